import math
import cadquery as cq
from OCP.gp import gp_GTrsf, gp_Mat
from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform

# =====================================================================
#  Bomb-carrying goblin figurine
#  character faces -Y, stands on Z=0, bombs strapped to its back (+Y)
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
H = 100.0                       # overall height (sole to helmet top)

# head / helmet
HEAD_C = (0.0, 0.0, 77.0)       # helmet spheroid centre
HEAD_R = (18.5, 22.5, 22.5)     # helmet semi-axes (X, Y, Z); Y == Z (spheroid about X)
CREST_W = 15.0                  # width of the raised helmet crest band
CREST_T = 1.2                   # crest height above helmet
FACE_C = (0.0, -12.0, 66.5)     # muzzle spheroid centre
FACE_A = 21.0                   # muzzle half-width (X)
FACE_RR = 13.0                  # muzzle radius about the X axis
GRIN_R = 25.0                   # radius of the grin arc
GRIN_Z = 59.5                   # lowest point of the grin (centre of the mouth)
# goggles
GOG_X = 13.5
GOG_Z = 77.5
GOG_Y0 = -15.0                  # back of goggle barrels
GOG_Y1 = -27.5                  # front face of goggles
GOG_RO = 7.6
GOG_RI = 5.4
# ears
EAR_A = (16.5, -6.0, 85.0)      # front-upper root corner (+X side)
EAR_B = (19.5, 5.0, 67.0)       # rear-lower root corner
EAR_TIP = (34.0, 12.0, 95.0)
EAR_T = 3.0

# torso (tapered barrel)
TORSO_Y = 3.0
TORSO_Z = (20.0, 54.0)
TORSO_RB = 12.5                 # bottom radius
TORSO_RT = 16.0                 # top radius
CHEST_TILT = 8.0               # chest plate leans forward at the top

# bombs
BIG_C = (0.0, 38.5, 38.0)
BIG_R = 27.0
SMALL_R = 15.5
SMALL_L = (-17.0, 31.0, 67.5)
SMALL_RC = (14.0, 31.0, 67.5)

# legs / feet
LEG_X = 16.5
FOOT_TOE_Y = -15.0
FOOT_HEEL_Y = 23.0
FOOT_W = 22.0
FOOT_H = 11.0

# arms
ARM_Y = 8.0
HAND_X = 43.0


# ---------------- helpers ----------------
def ellipsoid(c, rx, ry, rz, tilt_x=0.0):
    """ellipsoid = unit sphere scaled non-uniformly, optionally pitched about X"""
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(rx, 0, 0, 0, ry, 0, 0, 0, rz))
    sh = cq.Shape.cast(BRepBuilderAPI_GTransform(s.wrapped, g, True).Shape())
    w = cq.Workplane("XY").add(sh)
    if tilt_x:
        w = w.rotate((0, 0, 0), (1, 0, 0), tilt_x)
    return w.translate(c)


def scale_xyz(shape, sx, sy, sz):
    """non-uniform scaling (result is a B-spline solid)"""
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(sx, 0, 0, 0, sy, 0, 0, 0, sz))
    return cq.Shape.cast(BRepBuilderAPI_GTransform(shape.wrapped, g, True).Shape())


def spheroid(c, a, r, axis="X"):
    """spheroid: semi-axis a along `axis`, radius r around it"""
    if axis == "X":
        return ellipsoid(c, a, r, r)
    if axis == "Y":
        return ellipsoid(c, r, a, r)
    return ellipsoid(c, r, r, a)


def sphere(c, r):
    return cq.Workplane("XY").sphere(r).translate(c)


def box(c, sx, sy, sz, rot=None):
    b = cq.Workplane("XY").box(sx, sy, sz)
    if rot:
        for axis, ang in rot:
            b = b.rotate((0, 0, 0), axis, ang)
    return b.translate(c)


def _perp(d):
    a = cq.Vector(0, 0, 1) if abs(d.z) < 0.9 else cq.Vector(1, 0, 0)
    return d.cross(a).normalized()


def plane_at(p0, direction):
    d = cq.Vector(*direction).normalized()
    return cq.Plane(origin=p0, xDir=_perp(d), normal=d)


def cyl(p0, direction, r, h):
    return cq.Workplane(plane_at(p0, direction)).circle(r).extrude(h)


def slab(pts, n, t, off=0.0):
    """flat plate through 3D points (projected onto a common plane), thickness t along n"""
    p0 = pts[0]
    pts = [p - n * (p - p0).dot(n) for p in pts]
    w = cq.Workplane("XY").polyline([p.toTuple() for p in pts]).close().wires().val()
    sol = cq.Solid.extrudeLinear(cq.Face.makeFromWires(w), n * t)
    return cq.Workplane("XY").add(sol).translate((n * off).toTuple())


def ribbon(points, w=3.0, t=1.1):
    """crooked flat fuse: one flat strip per polyline segment"""
    out = []
    for i in range(len(points) - 1):
        a = cq.Vector(*points[i])
        b = cq.Vector(*points[i + 1])
        d = b - a
        L = d.Length
        dn = d.normalized()
        side = dn.cross(cq.Vector(0, 0, 1) if abs(dn.z) < 0.9 else cq.Vector(1, 0, 0)).normalized()
        if i % 2:
            side = (side + dn.cross(side) * 0.8).normalized()
        start = a - dn * 0.6
        out.append(cq.Workplane(cq.Plane(origin=start.toTuple(), xDir=side.toTuple(),
                                         normal=dn.toTuple()))
                   .rect(w, t).extrude(L + 1.2))
    return out


def fuse_cap(centre, radius, direction):
    """collar + 4 prongs on a bomb surface"""
    d = cq.Vector(*direction).normalized()
    c = cq.Vector(*centre)
    p = c + d * (radius - 1.5)
    cap = cyl(p.toTuple(), d.toTuple(), radius * 0.22, 3.2)
    pl = plane_at(p.toTuple(), d.toTuple())
    for k in range(4):
        ang = math.radians(45 + 90 * k)
        u = pl.xDir * math.cos(ang) + pl.yDir * math.sin(ang)
        q = c + (d * math.cos(0.32) + u * math.sin(0.32)).normalized() * (radius - 0.8)
        prong = (cq.Workplane(cq.Plane(origin=q.toTuple(), xDir=u.toTuple(),
                                       normal=(q - c).normalized().toTuple()))
                 .rect(radius * 0.32, radius * 0.14).extrude(1.8))
        cap = cap.union(prong)
    return cap


def safe_union(a, b):
    """boolean union with a sanity check; nudges b slightly if the kernel misbehaves"""
    va, vb = a.val().Volume(), b.val().Volume()
    for k in range(4):
        bb = b if k == 0 else b.translate((0.03 * k, 0.02 * k, -0.025 * k))
        u = a.union(bb)
        if len(u.solids().vals()) == 1 and u.val().Volume() >= max(va, vb) - 1e-3:
            return u
    return u


PARTS = []          # every feature solid; fused once at the end


def add(*ws):
    for w in ws:
        if isinstance(w, (list, tuple)):
            add(*w)
        else:
            PARTS.extend(w.solids().vals())


# =====================================================================
# HEAD
# =====================================================================
def helmet():
    """helmet spheroid (about X) with a raised crest band: one revolved profile of
    circular arcs (sphere radius R, crest radius R + CREST_T), then squeezed along X"""
    a, R = HEAD_R[0], HEAD_R[1]
    R2 = R + CREST_T
    xc = CREST_W / 2 * R / a                      # crest half-width before squeezing
    y_in = math.sqrt(R * R - xc * xc)
    y_out = math.sqrt(R2 * R2 - xc * xc)
    xm = (R + xc) / 2                             # arc mid-points on the plain helmet
    ym = math.sqrt(R * R - xm * xm)
    prof = (cq.Workplane("XY").moveTo(-R, 0)
            .threePointArc((-xm, ym), (-xc, y_in))
            .lineTo(-xc, y_out)
            .threePointArc((0, R2), (xc, y_out))      # crest
            .lineTo(xc, y_in)
            .threePointArc((xm, ym), (R, 0))
            .close())
    sol = prof.revolve(360, (-R, 0, 0), (R, 0, 0)).val()
    sol = scale_xyz(sol, a / R, 1.0, 1.0)
    return cq.Workplane("XY").add(sol.translate(cq.Vector(*HEAD_C)))


add(helmet())

# octagonal bolts on the helmet top
for sx in (-1, 1):
    d = cq.Vector(sx * 0.72, -0.33, 0.63).normalized()
    p = cq.Vector(sx * 11.5, HEAD_C[1] - 8.0, HEAD_C[2] + 14.0) - d * 1.0
    add(cq.Workplane(plane_at(p.toTuple(), d.toTuple())).polygon(8, 7.8).extrude(3.6))

# muzzle / jaw with wide cheeks; the grin is cut into it
face = spheroid(FACE_C, FACE_A, FACE_RR, "X")          # wide muzzle, brow and jaw in one
for sx in (-1, 1):
    face = safe_union(face, sphere((sx * 13.0, -8.0, 65.0), 8.5))   # cheeks


def crescent(cz, r, th, zlo, zhi):
    """thin spherical shell slice: its intersection with the muzzle is the grin line"""
    shell = sphere((0, -14.0, cz), r).cut(sphere((0, -14.0, cz + th), r - th * 0.15))
    return shell.intersect(box((0, -26, (zlo + zhi) / 2), 60, 14, zhi - zlo))


face = (face.cut(crescent(GRIN_Z + GRIN_R, GRIN_R, 1.6, GRIN_Z - 4.0, GRIN_Z + 11.0))
        .cut(crescent(GRIN_Z - 4.0 + GRIN_R, GRIN_R - 0.5, 0.8, GRIN_Z - 7.0, GRIN_Z + 4.0)))
add(face)

# nose
add(sphere((0, -25.0, 71.0), 2.8))

# layered neck scarf under the jaw (front edge drooping): rounded discs
for (yc, zc, rr, hh, tl) in ((-4.0, 53.0, 19.0, 4.5, 14.0), (-5.0, 49.5, 16.5, 3.5, 18.0)):
    add(cq.Workplane("XY").circle(rr).extrude(hh).translate((0, 0, -hh / 2))
        .edges().chamfer(hh * 0.4)
        .rotate((0, 0, 0), (1, 0, 0), tl).translate((0, yc, zc)))

# goggles: octagonal rims with recessed lenses
for sx in (-1, 1):
    L = GOG_Y0 - GOG_Y1
    wp = cq.Workplane(plane_at((sx * GOG_X, GOG_Y0, GOG_Z), (0, -1, 0)))
    gog = (wp.circle(GOG_RO - 1.0).extrude(L - 3.0)                    # barrel
           .faces("<Y").workplane().polygon(8, 2 * GOG_RO).extrude(3.0)   # rim
           .faces("<Y").workplane().hole(2 * GOG_RI, 1.2))              # recessed lens
    add(gog)
# strap: bridge between the goggles and an elliptic band around the helmet
add(box((0, -18.5, GOG_Z + 1.0), 14, 4, 3.5))
band = (cq.Workplane("XY").workplane(offset=GOG_Z - 1.0).center(0, HEAD_C[1])
        .ellipse(HEAD_R[0] + 1.0, HEAD_R[1] + 1.0).ellipse(HEAD_R[0] - 1.5, HEAD_R[1] - 1.5)
        .extrude(3.5))
add(band.intersect(box((0, 14.0, GOG_Z), 60, 52, 10)))


# ears: leaf blades rooted along the helmet side, tips up, out and back
def ear(sx):
    A = cq.Vector(sx * EAR_A[0], EAR_A[1], EAR_A[2])
    B = cq.Vector(sx * EAR_B[0], EAR_B[1], EAR_B[2])
    T = cq.Vector(sx * EAR_TIP[0], EAR_TIP[1], EAR_TIP[2])
    n = (A - B).cross(T - B).normalized()
    if n.x * sx < 0:
        n = n * -1

    def bulge(P, Q, away, k):
        e = (Q - P).normalized()
        p = n.cross(e)
        if p.dot(away - P) > 0:
            p = p * -1
        return P + (Q - P) * 0.5 + p * k

    U = bulge(A, T, B, 2.0)        # upper edge swell
    Lo = bulge(B, T, A, 2.5)       # lower edge lobe
    A2 = A + (A - B).normalized() * 1.5
    add(slab([A2, U, T, Lo, B], n, EAR_T, -EAR_T / 2))
    # inner fold ridge
    c = (A + B) * 0.5
    fold = [c + (A - c) * 0.5, T + (c - T) * 0.12, c + (B - c) * 0.5]
    add(slab(fold, n, 1.4, EAR_T / 2 - 0.2))
    if sx > 0:
        # earring: hoop threaded through the lower edge of the +X ear
        m = B + (T - B) * 0.3
        out = (m - (A + B) * 0.5)
        out = (out - n * out.dot(n)).normalized()
        c = m + out * 1.5
        e = (T - B).normalized()
        add(cq.Workplane(plane_at((c - e * 0.6).toTuple(), e.toTuple()))
            .circle(3.6).circle(2.5).extrude(1.2))


ear(1)
ear(-1)

# =====================================================================
# TORSO
# =====================================================================
add(cq.Workplane("XY").workplane(offset=TORSO_Z[0])
    .center(0, TORSO_Y).circle(TORSO_RB)
    .workplane(offset=TORSO_Z[1] - TORSO_Z[0]).circle(TORSO_RT).loft())
# trapezoidal chest plate
add(cq.Workplane("XZ").polyline([(-16, 49), (16, 49), (10.5, 27), (-10.5, 27)])
    .close().extrude(4.0).translate((0, -7.0, 0))
    .rotate((0, -7.0, 27), (1, -7.0, 27), CHEST_TILT))
add(box((0, -7.0, 51.5), 26, 8, 5))
# collar / scarf plates under the jaw
for sx in (-1, 1):
    add(box((sx * 14.5, -6.5, 52.4), 18, 16, 4,
            rot=[((0, 1, 0), sx * 18), ((0, 0, 1), sx * -15)]))
# waist band
add(cyl((0, TORSO_Y, 18.0), (0, 0, 1), 12.0, 4.0))
# harness strap over the shoulders to the bombs
add(box((0, 17.0, 50.0), 30, 14, 8))


# =====================================================================
# LEGS AND FEET
# =====================================================================
def leg(sx):
    x = sx * LEG_X
    # slanted hip block
    add(cq.Workplane("XY").box(13.0, 14.0, 11.0).edges("|Y").chamfer(2.0)
        .rotate((0, 0, 0), (0, 1, 0), sx * -22).rotate((0, 0, 0), (1, 0, 0), -10)
        .translate((x + sx * 1.0, 1.0, 26.0)))
    # piston rods between hip and ankle cuff
    for dx, dy in ((-4.0, 0.0), (-1.3, -1.0), (1.3, -1.0), (4.0, 0.0)):
        add(cyl((x + dx, 2.0 + dy, 14.0), (0, 0, 1), 1.0, 9.0))
    add(cyl((x, 4.5, 14.0), (0, 0, 1), 3.5, 9.0))
    # ankle cuff: thick elliptic slab tipped forward
    add(cq.Workplane("XY").ellipse(11.0, 10.0).extrude(5.0).edges().chamfer(1.0)
        .translate((0, 0, -2.5)).rotate((0, 0, 0), (1, 0, 0), -16)
        .translate((x, 0.5, 13.0)))
    # foot: domed toe cap with flat sole, plus a heel block
    add(spheroid((x, FOOT_TOE_Y + 15.0, 0.0), 15.0, FOOT_H, "Y")
        .intersect(box((x, 3.0, 10.0), 40, 60, 20)))
    add(box((x, FOOT_HEEL_Y - 8.0, 3.5), FOOT_W - 4, 16, 7))


leg(1)
leg(-1)


# =====================================================================
# ARMS
# =====================================================================
def arm(sx):
    y = ARM_Y
    add(box((sx * 24.0, y, 49.5), 13, 17, 6, rot=[((0, 1, 0), sx * -28)]))      # shoulder pad
    add(cyl((sx * 25.0, y, 49.0), (sx * 0.55, 0, -1), 4.2, 11.0))              # upper arm
    add(cq.Workplane(plane_at((sx * 20.0, y - 8.0, 47.0), (sx * 0.3, -1, 0.2)))
        .polygon(8, 6.5).extrude(3.0))                                          # shoulder bolt
    add(cq.Workplane("XY").polygon(6, 15.0).extrude(5.0).translate((0, 0, -2.5))
        .rotate((0, 0, 0), (0, 1, 0), sx * -30).translate((sx * 32.0, y, 41.0)))  # elbow ring
    add(cyl((sx * 32.0, y, 41.0), (sx * 0.6, 0, -1), 3.6, 9.0))                # forearm
    # big faceted gauntlet: block with a pyramidal (chamfered) lower end
    add(cq.Workplane("XY").box(12.0, 17.0, 19.0).edges("<Z").chamfer(5.2)
        .edges(">Z").chamfer(1.5)
        .rotate((0, 0, 0), (0, 1, 0), sx * -14)
        .translate((sx * HAND_X, y + 1.0, 29.0)))
    add(box((sx * 38.5, y, 39.0), 12, 17.5, 3.5, rot=[((0, 1, 0), sx * -22)]))  # cuff band
    # claw fingers hanging down on the inner side, plus a thumb
    for k in range(3):
        add(box((sx * 38.0, y - 5.0 + 5.0 * k, 19.5), 3.6, 3.6, 14.0,
                rot=[((0, 1, 0), sx * 12), ((1, 0, 0), 8 - 8 * k)]))
    add(box((sx * 36.0, y - 8.0, 23.0), 3.2, 3.2, 10.0, rot=[((1, 0, 0), 20)]))


arm(1)
arm(-1)

# =====================================================================
# BOMBS (one large, two small) with fuse caps and crooked fuses
# =====================================================================
add(sphere(BIG_C, BIG_R), sphere(SMALL_L, SMALL_R), sphere(SMALL_RC, SMALL_R))


def bomb_fuse(c, r, direction, pts, w=3.0):
    add(fuse_cap(c, r, direction))
    d = cq.Vector(*direction).normalized()
    p0 = cq.Vector(*c) + d * (r + 1.0)
    add(ribbon([p0.toTuple()] + pts, w=w))


bomb_fuse(BIG_C, BIG_R, (0.0, 0.76, 0.65),
          [(-5.5, 71.0, 60.0), (-11.0, 78.5, 61.5), (-13.0, 82.5, 56.0), (-14.0, 85.0, 47.0),
           (-18.0, 88.0, 45.5), (-22.0, 92.5, 43.0)])
bomb_fuse(SMALL_L, SMALL_R, (-0.70, 0.64, 0.32),
          [(-35.0, 47.0, 73.0), (-39.0, 48.5, 65.0), (-45.5, 50.0, 60.0)], 2.4)
bomb_fuse(SMALL_RC, SMALL_R, (0.40, 0.45, 0.80),
          [(20.5, 48.5, 84.5), (21.5, 54.0, 80.5), (22.0, 63.0, 76.5)], 2.4)

# =====================================================================
# single boolean fuse of all features
# =====================================================================
_fused = PARTS[0].fuse(*PARTS[1:]).clean()
if not (_fused.isValid() and len(_fused.Solids()) == 1):
    # fallback: plain sequential union (slower, but robust)
    _acc = cq.Workplane("XY").add(PARTS[0])
    for _p in PARTS[1:]:
        _acc = _acc.union(cq.Workplane("XY").add(_p))
    _fused = _acc.val()
result = cq.Workplane("XY").add(_fused)
